import cadquery as cq
from OCP.TopExp import TopExp
from OCP.TopAbs import TopAbs_EDGE, TopAbs_FACE
from OCP.TopTools import TopTools_IndexedDataMapOfShapeListOfShape
from OCP.BRepFilletAPI import BRepFilletAPI_MakeFillet

# ---------------- driving dimensions (mm) ----------------
H = 99.6           # overall height (bottom to top of hooks)
W = 105.0          # overall width along Y
T = 5.4            # frame bar thickness (along X)
GAP = 12.3         # clear gap between front and back frame
RAIL = 11.3        # side rail width (along Y) = hook width
BOT = 6.5          # bottom bar height
HF = 69.4          # front frame height
TOPF = 5.3         # front frame top bar height
HOOK_T = 5.5       # hook top thickness
TOPB_TOP = H - HOOK_T  # back frame top bar: top face (flush with hook underside)
TOPB = 5.6         # back frame top bar height
WIN_R = 5.3        # window corner radius
HOOK_X = 41.9      # overall depth (front face to hook tip outer face)
HOOK_TIP = 5.6     # hook tip thickness (X)
HOOK_DROP = 12.5   # hook tip length measured from top
R_EDGE = 1.0       # general rounding of convex edges
R_WIN = 1.0        # rounding of the window perimeter edges
R_HOOK_OUT = 2.5   # hook profile: outer top corner at the tip
R_HOOK_BACK = 1.6  # hook profile: outer top corner at the back
R_HOOK_TIP = 1.1   # hook profile: tip end corners
R_HOOK_IN = 1.8    # hook profile: inside corner at the back frame
R_HOOK_IN_TIP = 2.3  # hook profile: inside corner at the tip
R_NOTCH = 1.0      # where the back top bar runs into the hooks

XB = T + GAP       # back frame front face (x)


def frame(x0, height, top_bar):
    """Rectangular frame lying in YZ plane, thickness T along X, starting at x0."""
    outer = (
        cq.Workplane("YZ", origin=(x0, 0, 0))
        .center(0, height / 2.0)
        .rect(W, height)
        .extrude(T)
    )
    win_h = height - BOT - top_bar
    window = (
        cq.Workplane("YZ", origin=(x0 - 1, 0, 0))
        .center(0, BOT + win_h / 2.0)
        .sketch()
        .rect(W - 2 * RAIL, win_h)
        .vertices()
        .fillet(WIN_R)
        .finalize()
        .extrude(T + 2)
    )
    return outer.cut(window)


# front frame
front = frame(0.0, HF, TOPF)

# back frame (up to the top of its top bar)
back = frame(XB, TOPB_TOP, TOPB)

# hooks (J profile in XZ) at both Y ends
hook_prof = (
    cq.Workplane("XZ")
    .polyline(
        [
            (XB, TOPB_TOP - 1.0),
            (XB + T, TOPB_TOP - 1.0),
            (XB + T, H - HOOK_T),
            (HOOK_X - HOOK_TIP, H - HOOK_T),
            (HOOK_X - HOOK_TIP, H - HOOK_DROP),
            (HOOK_X, H - HOOK_DROP),
            (HOOK_X, H),
            (XB, H),
        ]
    )
    .close()
)
hook_solid = hook_prof.extrude(-RAIL)  # XZ normal is -Y, extrude(-d) goes +Y
hook_l = hook_solid.translate((0, -W / 2.0, 0))
hook_r = hook_solid.translate((0, W / 2.0 - RAIL, 0))

# bottom end bars joining the two frames
end_bar = cq.Workplane("XY").box(GAP, RAIL, BOT, centered=False)
end_l = end_bar.translate((T, -W / 2.0, 0))
end_r = end_bar.translate((T, W / 2.0 - RAIL, 0))

body = front.union(back).union(hook_l).union(hook_r).union(end_l).union(end_r)
solid = body.val()


def classify_edges(shp):
    """Return (convex_edges, concave_edges) of a solid (sharp edges only)."""
    emap = TopTools_IndexedDataMapOfShapeListOfShape()
    TopExp.MapShapesAndAncestors_s(shp.wrapped, TopAbs_EDGE, TopAbs_FACE, emap)
    convex, concave = [], []
    eps = 0.05
    for i in range(1, emap.Extent() + 1):
        e = cq.Edge(emap.FindKey(i))
        flist = list(emap.FindFromIndex(i))
        if len(flist) != 2:
            continue
        f1, f2 = cq.Face(flist[0]), cq.Face(flist[1])
        p = e.positionAt(0.5)
        n1 = f1.normalAt(p)
        n2 = f2.normalAt(p)
        d = n1 - n2
        if d.Length < 1e-3:
            continue  # tangent / smooth edge
        d = d.normalized()
        in1 = shp.isInside(p + d * eps, 1e-4)
        in2 = shp.isInside(p - d * eps, 1e-4)
        if not in1 and not in2:
            convex.append(e)
        elif in1 and in2:
            concave.append(e)
    return convex, concave


convex_edges, concave_edges = classify_edges(solid)


def near(a, b, tol=0.05):
    return abs(a - b) < tol


def edge_radius(e, convex):
    """Pick the rounding radius of an edge from where it sits on the part."""
    p = e.positionAt(0.5)
    t = e.tangentAt(0.5)
    along_y = abs(t.y) > 0.99
    in_hook = abs(p.y) > W / 2.0 - RAIL - 0.05
    if along_y and in_hook and p.z > H - HOOK_DROP - 0.1:
        # edges of the J-hook profile
        if near(p.x, HOOK_X) and near(p.z, H):
            return R_HOOK_OUT
        if near(p.x, XB) and near(p.z, H):
            return R_HOOK_BACK
        if near(p.z, H - HOOK_DROP):
            return R_HOOK_TIP
        if not convex and near(p.x, HOOK_X - HOOK_TIP):
            return R_HOOK_IN_TIP
        if not convex and near(p.x, XB + T):
            return R_HOOK_IN
    if not convex:
        # back top bar running into the side face of a hook
        if abs(t.x) > 0.99 and near(p.z, TOPB_TOP) and in_hook:
            return R_NOTCH
        return None
    # window perimeter edges of both frames
    if abs(t.x) < 1e-3 and abs(p.y) < W / 2.0 - RAIL + 0.05 and p.z > BOT - 0.05:
        if (near(p.x, 0.0) or near(p.x, T)) and p.z < HF - TOPF + 0.05:
            return R_WIN
        if (near(p.x, XB) or near(p.x, XB + T)) and p.z < TOPB_TOP - TOPB + 0.05:
            return R_WIN
    return R_EDGE


def rounded(shp, k=1.0):
    mk = BRepFilletAPI_MakeFillet(shp.wrapped)
    n = 0
    for e in convex_edges:
        r = edge_radius(e, True)
        if r:
            mk.Add(r * k, e.wrapped)
            n += 1
    for e in concave_edges:
        r = edge_radius(e, False)
        if r:
            mk.Add(r * k, e.wrapped)
            n += 1
    mk.Build()
    if not mk.IsDone():
        raise RuntimeError("fillet failed")
    return cq.Shape.cast(mk.Shape())


result = body
done = False
for k in (1.0, 0.9, 0.75, 0.5):
    try:
        s3 = rounded(solid, k)
        if s3.isValid():
            sols = s3.Solids()
            result = cq.Workplane("XY").newObject(sols if len(sols) == 1 else [s3])
            done = True
            break
    except Exception:
        pass

VIEW = {"azimuth": 45, "elevation": 26}
